import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 94.6          # tray length (Y)
W = 31.0          # tray width (X), open on +X side
H = 17.6          # wall height
HP = 22.2         # corner post height
TF = 3.2          # floor thickness
TW = 3.4          # -X side wall thickness
TE = 9.8          # end wall thickness at floor level
LIP = 13.0        # end-wall lip reach (from outer end face)
LIP_Z1 = 12.9     # lip underside lower height
LIP_Z2 = 16.9     # lip underside upper height
RC = 6.4          # big vertical corner radius at -X corners
CH_END = 8.0      # big chamfer on the outer top edge of the end walls
R_POSTBLEND = 3.0 # concave blend between end wall top and post
POST_W = 8.0      # post size in X
POST_L = 12.2     # post size in Y
POST_R = 1.3      # post vertical edge radius
POST_TOP_R = 0.6  # post top edge round
POST_OUT_R = 1.3  # post outer -X vertical edge round
POST_HOLE = 3.2   # post screw hole
POST_HOLE_CH = 0.6
POST_HOLE_BCH = 0.8 # chamfer at the bottom of the post holes
CUT_R = 16.4      # floor relief arc radius
CUT_OFF = 7.8     # arc centre beyond +X edge
POCKET_R = 1.5    # inner vertical corner radius of the pocket
END_R = 1.2       # round on the open-side end of the end walls
WALL_IN_CH = 0.9  # chamfer on inner top edge of -X wall
WALL_OUT_R = 0.8  # round on outer top edge of -X wall
BOT_CH = 0.4      # chamfer around the bottom

TAB_LEN = 35.2    # mounting tab length (-X)
TAB_W = 32.4      # tab width (Y) at the bottom
TAB_H = 11.8      # tab height
TAB_FLAT = 10.8   # tab top flat width
TAB_SIDE = 1.3    # vertical band at tab bottom
HOLE_X = (9.4, 25.0)  # hole distances from tray -X face
HOLE_D = 6.9
CBORE_D = 13.2
CBORE_DEPTH = 6.0


class BoxSel(cq.Selector):
    """select objects whose centre lies inside an axis aligned box"""

    def __init__(self, lo, hi):
        self.lo = lo
        self.hi = hi

    def filter(self, objs):
        out = []
        for o in objs:
            c = o.Center()
            p = (c.x, c.y, c.z)
            if all(self.lo[i] <= p[i] <= self.hi[i] for i in range(3)):
                out.append(o)
        return out


class FarY(cq.Selector):
    """select objects whose centre has |y| above a limit"""

    def __init__(self, lim):
        self.lim = lim

    def filter(self, objs):
        return [o for o in objs if abs(o.Center().y) > self.lim]


def sel_and(*sels):
    out = sels[0]
    for s in sels[1:]:
        out = cq.selectors.AndSelector(out, s)
    return out


def try_fillet(wp, sel, r, chamfer=False):
    """fillet (or chamfer) the selected edges, keep the part unchanged on failure"""
    try:
        edges = wp.edges(sel)
        if len(edges.vals()) == 0:
            return wp
        out = edges.chamfer(r) if chamfer else edges.fillet(r)
        if out.val().isValid():
            return out
    except Exception:
        pass
    return wp


ZSEL = cq.selectors.StringSyntaxSelector("|Z")

# ---------------- tray envelope ----------------
# plan outline (big radius on the -X corners), full post height
plan = (cq.Workplane("XY")
        .box(W, L, HP, centered=(False, True, False))
        .edges("|Z and <X").fillet(RC)
        .edges("|Z and >X").fillet(POST_R))

# side profile of the walled part: end walls chamfered on the outside top
side_a = (cq.Workplane("YZ").workplane(offset=-1)
          .rect(L, H, centered=(True, False))
          .extrude(W - POST_W + 1)
          .edges("|X and >Z").chamfer(CH_END))

# side profile under the posts: square, posts rise to HP at both ends
side_b = (cq.Workplane("YZ").workplane(offset=W - POST_W)
          .polyline([(-L / 2, 0), (L / 2, 0), (L / 2, HP), (L / 2 - POST_L, HP),
                     (L / 2 - POST_L, H), (-L / 2 + POST_L, H),
                     (-L / 2 + POST_L, HP), (-L / 2, HP)])
          .close().extrude(POST_W + 1))

body = plan.intersect(side_a.union(side_b))

# concave blend where the end wall top / chamfer meets the posts, then
# round the outer -X edge of each post into the end face
body = try_fillet(body, BoxSel((W - POST_W - 0.05, -L / 2 + 0.1, H - CH_END - 0.5),
                               (W - POST_W + 0.05, L / 2 - 0.1, H + 0.05)), R_POSTBLEND)
body = try_fillet(body, sel_and(BoxSel((W - POST_W - 0.1, -L, H - CH_END), (W - POST_W + 0.1, L, HP)),
                                FarY(L / 2 - 0.05)), POST_OUT_R)

# post vertical edges on the inner side
body = try_fillet(body, sel_and(ZSEL, BoxSel((W - 0.05, -L / 2 + 0.5, H + 0.5),
                                              (W + 0.05, L / 2 - 0.5, HP))), POST_R)
body = try_fillet(body, sel_and(ZSEL, BoxSel((W - POST_W - 0.05, -L / 2 + 0.5, H + 0.5),
                                              (W - POST_W + 0.05, L / 2 - 0.5, HP))), POST_R)

# round the top edges of the posts
body = try_fillet(body, BoxSel((W - POST_W - 0.1, -L, HP - 0.01), (W + 0.1, L, HP + 0.01)),
                  POST_TOP_R)

# ---------------- inner pocket with lipped end walls ----------------
yi = L / 2 - TE
yl = L / 2 - LIP
pocket_pts = [(-yi, TF), (yi, TF), (yi, LIP_Z1), (yl, LIP_Z2), (yl, H + 1),
              (-yl, H + 1), (-yl, LIP_Z2), (-yi, LIP_Z1)]
pocket = (cq.Workplane("YZ").workplane(offset=TW)
          .polyline(pocket_pts).close().extrude(W + 2 - TW))
body = body.cut(pocket)

# inner corners where the side wall meets the end walls
body = try_fillet(body, sel_and(ZSEL, BoxSel((TW - 0.05, -L, TF + 0.1), (TW + 0.05, L, LIP_Z1)),
                               FarY(L / 4)), POCKET_R)

# rounded open-side ends of the end walls
body = try_fillet(body, sel_and(ZSEL, BoxSel((W - 0.05, -yi - 0.05, TF), (W + 0.05, yi + 0.05, LIP_Z1))),
                  END_R)

# small round on the outer top edge of the side wall
wall_rd = (cq.Workplane("XZ").workplane(offset=-(L / 2 - CH_END + WALL_OUT_R))
           .moveTo(-1, H - WALL_OUT_R).lineTo(0, H - WALL_OUT_R)
           .threePointArc((WALL_OUT_R * (1 - 0.7071068), H - WALL_OUT_R * (1 - 0.7071068)),
                          (WALL_OUT_R, H))
           .lineTo(WALL_OUT_R, H + 1).lineTo(-1, H + 1).close()
           .extrude(L - 2 * (CH_END - WALL_OUT_R)))
body = body.cut(wall_rd)

# chamfer on the inner top edge of the side wall
wall_ch = (cq.Workplane("XZ").workplane(offset=-yl)
           .polyline([(TW - 0.01, H - WALL_IN_CH), (TW + 0.5, H - WALL_IN_CH), (TW + 0.5, H + 1),
                      (TW - WALL_IN_CH - 1, H + 1), (TW - WALL_IN_CH, H)])
           .close().extrude(2 * yl))
body = body.cut(wall_ch)

# floor relief arc on the open side
arc_cut = (cq.Workplane("XY").center(W + CUT_OFF, 0)
           .circle(CUT_R).extrude(H + 5).translate((0, 0, -1)))
body = body.cut(arc_cut)

# post screw holes (through) with a small lead-in chamfer
for s in (1, -1):
    cx, cy = W - POST_W / 2, s * (L / 2 - POST_L / 2)
    hole = (cq.Workplane("XY").center(cx, cy)
            .circle(POST_HOLE / 2).extrude(HP + 2).translate((0, 0, -1)))
    cone = cq.Solid.makeCone(POST_HOLE / 2, POST_HOLE / 2 + POST_HOLE_CH + 1.0,
                             POST_HOLE_CH + 1.0,
                             pnt=cq.Vector(cx, cy, HP - POST_HOLE_CH))
    cone_b = cq.Solid.makeCone(POST_HOLE / 2 + POST_HOLE_BCH + 1.0, POST_HOLE / 2,
                               POST_HOLE_BCH + 1.0, pnt=cq.Vector(cx, cy, -1.0))
    body = (body.cut(hole).cut(cq.Workplane("XY").add(cone))
            .cut(cq.Workplane("XY").add(cone_b)))

# ---------------- mounting tab ----------------
tw2 = TAB_W / 2
fw2 = TAB_FLAT / 2
tab_pts = [(-tw2, 0), (tw2, 0), (tw2, TAB_SIDE), (fw2, TAB_H),
           (-fw2, TAB_H), (-tw2, TAB_SIDE)]
tab = (cq.Workplane("YZ").workplane(offset=0.5)
       .polyline(tab_pts).close().extrude(-(TAB_LEN + 0.5)))
for hx in HOLE_X:
    thru = (cq.Workplane("XY").center(-hx, 0).circle(HOLE_D / 2)
            .extrude(TAB_H + 2).translate((0, 0, -1)))
    cb = (cq.Workplane("XY").center(-hx, 0).circle(CBORE_D / 2)
          .extrude(CBORE_DEPTH + 5).translate((0, 0, TAB_H - CBORE_DEPTH)))
    tab = tab.cut(thru).cut(cb)

result = body.union(tab).clean()

# small chamfer around the bottom outline
try:
    bottom = result.faces("<Z").val()
    outer = bottom.outerWire().Edges()
    ch = result.newObject(outer).chamfer(BOT_CH)
    if ch.val().isValid():
        result = ch
except Exception:
    pass
